"""Snap-in end cap / clip plug.

A vertical prism with a chevron-shaped plan (front V, rounded side corners,
concave back), a top that is flat at the front and rolls down towards the
back with a small ridge at the front tip, three clip tabs at the bottom (two
on the front faces, one at the back) and a short conical spigot underneath.
All dimensions in millimetres; +Z up, the V tip points to -Y.
"""
import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ====================== driving dimensions ======================
# --- plan (XY) outline of the body ---
W_HALF = 20.0             # half width (extreme x of the side corners)
Y_TIP = -13.79            # front V tip (sharp corner, before rounding)
FRONT_SLOPE = 0.361       # dy/d|x| of the two front faces (~19.9 deg)
SIDE_PT = (-18.42, 1.55)  # a point on the left rear-side face
SIDE_SLOPE = 0.978        # dy/dx of the left rear-side face (~44.4 deg)
BACK_R = 28.0             # radius of the concave back face
BACK_Y = 10.78            # back face position on the centre line
R_TIP = 3.0               # vertical round on the front crease
R_BACKC = 5.0             # vertical round on the two back corners
# (the side-corner round is derived so that the body is exactly 2*W_HALF wide)

# --- top surface: profile in the YZ plane, extruded along X ---
Z_FLAT = 43.3             # height of the flat front part of the top
Y_A = -5.14               # where the top starts to roll down
R1 = 14.5                 # roll-over radius
TOP_SLOPE = 0.34          # slope (dz/dy) of the rear part of the top
NOSE_H = 1.10             # height of the small ridge at the front tip
NOSE_GX = 0.013           # ridge flank slopes
NOSE_GY = 0.18

R_TOP = 1.7               # round on the top perimeter
R_BOT = 1.2               # round on the bottom perimeter

# --- clip tabs ---
TAB_H = 14.6              # tab height (from the bottom face)
TAB_R = 1.3               # round on the tab tops
FT_OUT = 12.78            # |x| of the outer side of the front tabs
FT_IN = 8.9               # |x| where the inner bevel leaves the tab nose
FT_Y = -13.9              # front face of the front tabs
FT_BEVEL = math.radians(38.0)   # inner bevel of the front tabs
FT_TAPER = math.radians(10.0)   # taper of the outer side of the front tabs
FT_R = 1.5                # round on the front-tab nose
BT_W = 5.9                # back tab width at the body
BT_Y = 14.2               # back tab end face
BT_TAPER = math.radians(20.6)   # side taper of the back tab
BT_R = 1.1                # round on the back-tab nose

# --- bottom spigot (short cone frustum) ---
DISC_R = 10.85            # radius where it meets the body
DISC_R_BOT = 9.0          # radius at the bottom face
DISC_H = 1.94             # height below the body
DISC_Y = -1.77            # centre offset along y
DISC_FIL = 0.5            # round on the bottom edge


# ====================== small 2D helpers ======================
def unit(v):
    l = math.hypot(v[0], v[1])
    return (v[0] / l, v[1] / l)


def line_x(p1, d1, p2, d2):
    """intersection of the lines p1 + t d1 and p2 + s d2"""
    det = d1[0] * (-d2[1]) - d1[1] * (-d2[0])
    rx, ry = p2[0] - p1[0], p2[1] - p1[1]
    t = (rx * (-d2[1]) - ry * (-d2[0])) / det
    return (p1[0] + t * d1[0], p1[1] + t * d1[1])


def fillet_ll(P, da, db, r):
    """round of radius r between the rays P + t*da and P + t*db -> (tangent a, arc mid, tangent b)"""
    da, db = unit(da), unit(db)
    ang = math.acos(da[0] * db[0] + da[1] * db[1])
    t = r / math.tan(ang / 2)
    bis = unit((da[0] + db[0], da[1] + db[1]))
    d = r / math.sin(ang / 2)
    c = (P[0] + bis[0] * d, P[1] + bis[1] * d)
    ta = (P[0] + da[0] * t, P[1] + da[1] * t)
    tb = (P[0] + db[0] * t, P[1] + db[1] * t)
    mid = (c[0] - bis[0] * r, c[1] - bis[1] * r)
    return ta, mid, tb


def mx(p):
    return (-p[0], p[1])


# ====================== plan outline ======================
dL1 = unit((-1.0, FRONT_SLOPE))   # front-left face, from the tip outwards
dL2 = unit((1.0, SIDE_SLOPE))     # left rear-side face, towards the back
tip = (0.0, Y_TIP)
PL = line_x(tip, dL1, SIDE_PT, dL2)          # sharp left corner

# side corner round: chosen so that its extreme x is -W_HALF
va = unit((tip[0] - PL[0], tip[1] - PL[1]))
ang = math.acos(va[0] * dL2[0] + va[1] * dL2[1])
bis = unit((va[0] + dL2[0], va[1] + dL2[1]))
R_SIDE = (-W_HALF - PL[0]) / (bis[0] / math.sin(ang / 2) - 1.0)
s_ta, s_mid, s_tb = fillet_ll(PL, va, dL2, R_SIDE)

# front crease round
t_ta, t_mid, t_tb = fillet_ll(tip, unit((1.0, FRONT_SLOPE)), unit((-1.0, FRONT_SLOPE)), R_TIP)

# back corner round: tangent to the rear-side face and (externally) to the concave back circle
C0 = (0.0, BACK_Y + BACK_R)
n_in = unit((dL2[1], -dL2[0]))               # inward normal of the left rear-side face
bx = SIDE_PT[0] + R_BACKC * n_in[0] - C0[0]
by = SIDE_PT[1] + R_BACKC * n_in[1] - C0[1]
qb = 2 * (bx * dL2[0] + by * dL2[1])
qc = bx * bx + by * by - (BACK_R + R_BACKC) ** 2
cands = []
for t in ((-qb + math.sqrt(qb * qb - 4 * qc)) / 2, (-qb - math.sqrt(qb * qb - 4 * qc)) / 2):
    cands.append((SIDE_PT[0] + t * dL2[0] + R_BACKC * n_in[0],
                  SIDE_PT[1] + t * dL2[1] + R_BACKC * n_in[1]))
Fc = min(cands, key=lambda f: f[1])          # centre of the back-corner round
b_tl = (Fc[0] - R_BACKC * n_in[0], Fc[1] - R_BACKC * n_in[1])        # tangent on the side face
kk = BACK_R / (BACK_R + R_BACKC)
b_tc = (C0[0] + (Fc[0] - C0[0]) * kk, C0[1] + (Fc[1] - C0[1]) * kk)  # tangent on the back arc
mdir = unit((b_tl[0] + b_tc[0] - 2 * Fc[0], b_tl[1] + b_tc[1] - 2 * Fc[1]))
b_mid = (Fc[0] + mdir[0] * R_BACKC, Fc[1] + mdir[1] * R_BACKC)

plan = (
    cq.Workplane("XY")
    .moveTo(*t_tb)
    .lineTo(*s_ta)
    .threePointArc(s_mid, s_tb)                  # left side corner
    .lineTo(*b_tl)
    .threePointArc(b_mid, b_tc)                  # back-left corner
    .threePointArc((0.0, BACK_Y), mx(b_tc))      # concave back
    .threePointArc(mx(b_mid), mx(b_tl))          # back-right corner
    .lineTo(*mx(s_tb))
    .threePointArc(mx(s_mid), mx(s_ta))          # right side corner
    .lineTo(*t_ta)
    .threePointArc(t_mid, t_tb)                  # front crease
    .close()
)
prism = plan.extrude(Z_FLAT + 6.0)

# ====================== top surface ======================
TH1 = math.atan(TOP_SLOPE)
y1 = Y_A + R1 * math.sin(TH1)
z1 = Z_FLAT - R1 * (1 - math.cos(TH1))
m1 = (Y_A + R1 * math.sin(TH1 / 2), Z_FLAT - R1 + R1 * math.cos(TH1 / 2))
Y_END = 20.0
z_end = z1 - TOP_SLOPE * (Y_END - y1)
keep = (
    cq.Workplane("YZ", origin=(-30, 0, 0))
    .moveTo(-25.0, -10)
    .lineTo(-25.0, Z_FLAT)
    .lineTo(Y_A, Z_FLAT)
    .threePointArc(m1, (y1, z1))                 # convex roll-over
    .lineTo(Y_END, z_end)                        # straight run-down to the back
    .lineTo(Y_END, -10)
    .close()
    .extrude(60)
)
body = prism.intersect(keep)

# small ridge at the front tip: two planes through the raised tip point
Z_TIP = Z_FLAT + NOSE_H
above = None
for sgn in (-1, 1):
    nrm = cq.Vector(sgn * NOSE_GX, NOSE_GY, 1.0)
    wp = cq.Workplane(cq.Plane(origin=(0, Y_TIP, Z_TIP), xDir=(1, 0, -sgn * NOSE_GX), normal=nrm))
    blk = wp.rect(200, 200).extrude(100)          # half space above the flank plane
    above = blk if above is None else above.union(blk)
nose_len = NOSE_H / NOSE_GY + 1.0
nose = (prism.cut(above)
        .intersect(cq.Workplane("XY").box(100, nose_len + 5, 10, centered=(True, False, False))
                   .translate((0, Y_TIP - 5, Z_FLAT - 0.5))))
body = body.union(nose)

# round the top perimeter (edges shared with the vertical side faces)
solid = body.val()
perim = []
for f in solid.Faces():
    if abs(f.normalAt(f.Center()).z) < 0.3:
        perim += [e for e in f.Edges() if e.Center().z > 30]
body = cq.Workplane("XY").add(solid.fillet(R_TOP, perim))


# ====================== clip tabs ======================
def front_tab(sgn):
    yb = -6.0                                       # buried end inside the body
    y_join = Y_TIP + FRONT_SLOPE * FT_OUT           # outer side meets the front face
    x_of = FT_OUT - (y_join - FT_Y) * math.tan(FT_TAPER)
    xin_back = FT_IN - (yb - FT_Y) * math.tan(FT_BEVEL)
    pts = [(x_of, FT_Y), (FT_IN, FT_Y), (xin_back, yb), (FT_OUT, yb), (FT_OUT, y_join)]
    t = cq.Workplane("XY").polyline([(sgn * x, y) for x, y in pts]).close().extrude(TAB_H)
    t = t.edges("|Z").edges(cq.selectors.BoxSelector((-30, FT_Y - 0.1, -1), (30, FT_Y + 0.1, 50))).fillet(FT_R)
    return t.faces(">Z").edges().fillet(TAB_R)


def back_tab():
    yb = BACK_Y - 3.0                               # buried end inside the body
    y0 = BACK_Y + 0.15
    hw_end = BT_W / 2 - (BT_Y - y0) * math.tan(BT_TAPER)
    hw_b = BT_W / 2 + (y0 - yb) * math.tan(BT_TAPER)
    pts = [(-hw_b, yb), (hw_b, yb), (hw_end, BT_Y), (-hw_end, BT_Y)]
    t = cq.Workplane("XY").polyline(pts).close().extrude(TAB_H)
    t = t.edges("|Z").edges(cq.selectors.BoxSelector((-30, BT_Y - 0.1, -1), (30, BT_Y + 0.1, 50))).fillet(BT_R)
    return t.faces(">Z").edges().fillet(TAB_R)


for t in (front_tab(-1), front_tab(1), back_tab()):
    body = body.union(t)
body = body.faces("<Z").edges().fillet(R_BOT)

# ====================== bottom spigot ======================
spigot = (
    cq.Workplane("XZ")
    .polyline([(0, 0.6), (DISC_R - 0.6, 0.6), (DISC_R - 0.6, 0.0), (DISC_R, 0.0),
               (DISC_R_BOT, -DISC_H), (0, -DISC_H)])
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .translate((0, DISC_Y, 0))
)
spigot = spigot.faces("<Z").edges().fillet(DISC_FIL)
body = body.union(spigot)

result = body
